import math
import cadquery as cq

# Square grid frame plate (3 x 3 openings, enlarged centre opening) with an
# upstanding flange behind each outer edge, cylindrical lobes with blind holes
# at the flange ends, bolt pads on the back face and engraved X markings.
# Plate lies in the world XZ plane (front face at Y=0), flanges point to +Y.

# ---------------- driving dimensions (mm) ----------------
HALF = 115.0          # half of the plate outer size (square)
T = 4.7               # plate thickness
OUTER_W = 16.0        # outer frame bar width  -> inner edge at HALF-OUTER_W
BAR_IN = 25.0         # inner grid bar, inner edge offset from centre
BAR_OUT = 48.5        # inner grid bar, outer edge offset from centre
BAR_END = 95.0        # outer bars stop here (open corners)
CORNER_R = 1.5        # corner radius of the openings

CEN_HALF = 31.5       # half size of the enlarged centre opening
CEN_DISC_R = 7.0      # material discs left in the centre-opening corners

EAR_POS = 46.0        # ear / lobe position along each edge
EAR_R = 5.5           # lobe radius
LOBE_HOLE_D = 2.5     # blind hole in the lobes
LOBE_HOLE_DEPTH = 8.0

FL_DEPTH = 29.0       # flange depth behind the front face
FL_HALF = 57.5        # flange half length
FL_TH = 4.7           # flange wall thickness (in plane of plate)
FL_ROUND = 8.5        # convex round at the back corners of a flange
FL_FILLET = 8.0       # concave fillet where a flange meets the plate
EAR_C = HALF - FL_TH / 2.0   # lobe axis distance from centre (mid-wall of flange)

PAD_H = 4.0           # pad height on the back face
PAD_IN = 22.0         # inner (4-hole) pad size
PAD_OUT_L = 23.5      # outer (2-hole) pad length along the bar
PAD_R = 4.5
HOLE_D = 3.5
HOLE_SP = 11.5        # hole spacing in the pads

MARK_S = 18.0         # engraved 'X in a box' marking size
MARK_W = 1.2          # groove width of the marking
MARK_DEPTH = 0.6
MARK_IN = 64.0        # marking centre when near the grid node
MARK_OUT = 84.0       # marking centre when near the outer frame
EDGE_R = 1.0          # small rounds on bar ends and ear roots

INNER = HALF - OUTER_W            # inner edge of outer bars
NODE = (BAR_IN + BAR_OUT) / 2.0   # inner grid line position
PAD_OUT_W = HALF - FL_TH - INNER  # outer pad width (bar inner edge to flange)
PAD_OUT_C = INNER + PAD_OUT_W / 2.0

# ---------------- plate (built in local XY, thickness along +Z) ----------------
plate = cq.Workplane("XY").rect(2 * HALF, 2 * HALF).extrude(T)

# open corners between the outer bars
corner_sz = HALF - BAR_END
for sx in (-1, 1):
    for sy in (-1, 1):
        c = (cq.Workplane("XY")
             .center(sx * (BAR_END + corner_sz / 2.0), sy * (BAR_END + corner_sz / 2.0))
             .rect(corner_sz, corner_sz).extrude(T))
        plate = plate.cut(c)

# eight regular openings
def span(i):
    if i == 0:
        return (-BAR_IN, BAR_IN)
    return (BAR_OUT, INNER) if i > 0 else (-INNER, -BAR_OUT)

for i in (-1, 0, 1):
    for j in (-1, 0, 1):
        if i == 0 and j == 0:
            continue
        x0, x1 = span(i)
        y0, y1 = span(j)
        op = (cq.Workplane("XY").center((x0 + x1) / 2, (y0 + y1) / 2)
              .rect(x1 - x0, y1 - y0).extrude(T)
              .edges("|Z").fillet(CORNER_R))
        plate = plate.cut(op)

# enlarged centre opening with material discs left in its corners
cen = cq.Workplane("XY").rect(2 * CEN_HALF, 2 * CEN_HALF).extrude(T)
for sx in (-1, 1):
    for sy in (-1, 1):
        disc = (cq.Workplane("XY").center(sx * CEN_HALF, sy * CEN_HALF)
                .circle(CEN_DISC_R).extrude(T))
        cen = cen.cut(disc)
plate = plate.cut(cen)


def fillet_vertical_edges(wp, pts, r, tol=0.3):
    """Round the edges parallel to local Z that pass through the given (x, y) points."""
    solid = wp.val()
    sel = []
    for e in solid.Edges():
        p0 = e.startPoint()
        p1 = e.endPoint()
        if abs(p0.x - p1.x) > 1e-6 or abs(p0.y - p1.y) > 1e-6:
            continue
        for (px, py) in pts:
            if abs(p0.x - px) < tol and abs(p0.y - py) < tol:
                sel.append(e)
                break
    if not sel:
        return wp
    return cq.Workplane("XY").add(solid.fillet(r, sel))


# small rounds on the free ends of the outer bars
bar_end_pts = []
for sx in (-1, 1):
    for sy in (-1, 1):
        bar_end_pts += [(sx * BAR_END, sy * HALF), (sx * BAR_END, sy * INNER),
                        (sx * HALF, sy * BAR_END), (sx * INNER, sy * BAR_END)]
plate = fillet_vertical_edges(plate, bar_end_pts, EDGE_R)

# blend the corner discs of the centre opening into its straight sides
cd = CEN_HALF - CEN_DISC_R
disc_pts = []
for sx in (-1, 1):
    for sy in (-1, 1):
        disc_pts += [(sx * CEN_HALF, sy * cd), (sx * cd, sy * CEN_HALF)]
plate = fillet_vertical_edges(plate, disc_pts, 1.5)

# ---------------- one edge flange (top edge, +Y local), then rotate ----------------
def edge_flange():
    L, Rf, Rc, D = FL_HALF, FL_FILLET, FL_ROUND, FL_DEPTH
    # profile in local (x, z) plane; sketch on a plane whose local y = z
    pl = cq.Plane(origin=(0, HALF, 0), xDir=(1, 0, 0), normal=(0, -1, 0))
    # smooth S-shaped flange end (single spline edge): concave blend into the
    # plate back face, straight flank, convex round into the flange back face
    mid_y = (T + Rf + D - Rc) / 2.0
    prof = (cq.Workplane(pl)
            .moveTo(-L - Rf, 0)
            .lineTo(L + Rf, 0)
            .lineTo(L + Rf, T)
            .spline([(L, mid_y), (L - Rc, D)],
                    tangents=[(-1, 0), (0, 1), (-1, 0)], includeCurrent=True)
            .lineTo(-L + Rc, D)
            .spline([(-L, mid_y), (-L - Rf, T)],
                    tangents=[(-1, 0), (0, -1), (-1, 0)], includeCurrent=True)
            .close()
            .extrude(FL_TH))
    fl = prof
    # lobes (cylinders along the depth) at the ear positions
    for sx in (-1, 1):
        lobe = (cq.Workplane("XY").center(sx * EAR_POS, EAR_C)
                .circle(EAR_R).extrude(D))
        clip = (cq.Workplane("XY").center(sx * EAR_POS, HALF - FL_TH + 10.0)
                .rect(4 * EAR_R, 20.0).extrude(D))
        fl = fl.union(lobe.intersect(clip))
    return fl

flange = edge_flange()
body = plate
for ang in (0, 90, 180, 270):
    body = body.union(flange.rotate((0, 0, 0), (0, 0, 1), ang))

# small rounds where the lobes (ears) run into the outer edge faces
ear_dx = math.sqrt(EAR_R ** 2 - (HALF - EAR_C) ** 2)
ear_pts = []
for s in (-1, 1):
    for side in (-1, 1):
        for d in (-ear_dx, ear_dx):
            ear_pts.append((s * EAR_POS + d, side * HALF))
            ear_pts.append((side * HALF, s * EAR_POS + d))
body = fillet_vertical_edges(body, ear_pts, EDGE_R)

# ---------------- pads on the back face ----------------
pads = None
def add(a, b):
    return b if a is None else a.union(b)

for sx in (-1, 1):
    for sy in (-1, 1):
        p = (cq.Workplane("XY").workplane(offset=T).center(sx * NODE, sy * NODE)
             .rect(PAD_IN, PAD_IN).extrude(PAD_H).edges("|Z").fillet(PAD_R))
        pads = add(pads, p)
for s in (-1, 1):
    for side in (-1, 1):
        # pads on top / bottom bars: square against the flange, rounded towards the grid
        p = (cq.Workplane("XY").workplane(offset=T).center(s * NODE, side * PAD_OUT_C)
             .rect(PAD_OUT_L, PAD_OUT_W).extrude(PAD_H))
        p = fillet_vertical_edges(p, [(s * NODE - PAD_OUT_L / 2, side * INNER),
                                      (s * NODE + PAD_OUT_L / 2, side * INNER)], PAD_R)
        pads = add(pads, p)
        # pads on left / right bars
        p = (cq.Workplane("XY").workplane(offset=T).center(side * PAD_OUT_C, s * NODE)
             .rect(PAD_OUT_W, PAD_OUT_L).extrude(PAD_H))
        p = fillet_vertical_edges(p, [(side * INNER, s * NODE - PAD_OUT_L / 2),
                                      (side * INNER, s * NODE + PAD_OUT_L / 2)], PAD_R)
        pads = add(pads, p)
body = body.union(pads)

# ---------------- holes ----------------
hs = HOLE_SP / 2.0
pts = []
for sx in (-1, 1):
    for sy in (-1, 1):
        for dx in (-hs, hs):
            for dy in (-hs, hs):
                pts.append((sx * NODE + dx, sy * NODE + dy))
for s in (-1, 1):
    for side in (-1, 1):
        for d in (-hs, hs):
            pts.append((s * NODE + d, side * PAD_OUT_C))
            pts.append((side * PAD_OUT_C, s * NODE + d))
holes = (cq.Workplane("XY").workplane(offset=-1).pushPoints(pts)
         .circle(HOLE_D / 2.0).extrude(T + PAD_H + 2))
body = body.cut(holes)

# blind holes in the lobes, from the front and from the back
lp = []
for s in (-1, 1):
    lp += [(s * EAR_POS, EAR_C), (s * EAR_POS, -EAR_C), (EAR_C, s * EAR_POS), (-EAR_C, s * EAR_POS)]
lh_front = (cq.Workplane("XY").workplane(offset=-1).pushPoints(lp)
            .circle(LOBE_HOLE_D / 2.0).extrude(LOBE_HOLE_DEPTH + 1))
lh_back = (cq.Workplane("XY").workplane(offset=FL_DEPTH - LOBE_HOLE_DEPTH).pushPoints(lp)
           .circle(LOBE_HOLE_D / 2.0).extrude(LOBE_HOLE_DEPTH + 1))
body = body.cut(lh_front).cut(lh_back)

# ---------------- engraved 'X in a box' markings on the grid arms (back face) ----------------
def x_mark(cx, cy):
    inner = MARK_S - 2 * MARK_W
    wp = cq.Workplane("XY").workplane(offset=T - MARK_DEPTH)
    frame = wp.center(cx, cy).rect(MARK_S, MARK_S).rect(inner, inner).extrude(MARK_DEPTH + 1)
    cross = None
    for ang in (45, -45):
        bar = (cq.Workplane("XY").workplane(offset=T - MARK_DEPTH)
               .transformed(offset=(cx, cy, 0), rotate=(0, 0, ang))
               .rect(inner * 1.5, MARK_W).extrude(MARK_DEPTH + 1))
        cross = bar if cross is None else cross.union(bar)
    clip = (cq.Workplane("XY").workplane(offset=T - MARK_DEPTH).center(cx, cy)
            .rect(inner, inner).extrude(MARK_DEPTH + 1))
    return frame.union(cross.intersect(clip))

# pinwheel arrangement (world x, world z); local y = -world z
mark_world = [(NODE, MARK_OUT), (-NODE, MARK_IN), (MARK_IN, NODE), (-MARK_OUT, NODE),
              (MARK_OUT, -NODE), (-MARK_IN, -NODE), (NODE, -MARK_IN), (-NODE, -MARK_OUT)]
marks = None
for (wx, wz) in mark_world:
    m = x_mark(wx, -wz)
    marks = m if marks is None else marks.union(m)
body = body.cut(marks)

# ---------------- orient: plate in world XZ, flanges toward +Y ----------------
result = body.rotate((0, 0, 0), (1, 0, 0), -90)

VIEW = {"azimuth": 45, "elevation": 26}
